import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Bear-head shaped jelly / cake mould, modelled upside-down:
# flat base plate on top, domed wall flaring out down to the open rim (z = 0).
HEAD_R = 53.1          # head lobe radius at the rim (circle)
EAR_CX = 24.25         # ear centre offset in X (+/-)
EAR_CY = 31.55         # ear centre offset in Y
EAR_A = 34.7           # ear ellipse semi-axis along its tilt direction
EAR_B = 31.15          # ear ellipse minor semi-axis
EAR_TILT = 68.1        # ear major-axis tilt from X axis (deg), points at head

WALL_H = 23.0          # height of the curved wall (rim -> base plate)
WALL_INSET = 9.4       # horizontal inset of the wall top relative to the rim
ARC_DROP = 1.7         # wall arc centre lies this far below the rim plane
WALL_T = 2.4           # wall thickness
BASE_T = 2.5           # flat base plate thickness
BASE_OVERHANG = 2.35   # base plate overhang past the wall top

EPS = 1.0              # construction margin for the cutting tools
OVL = 0.1              # overlap of the relief bosses into their support

# face relief hanging from the inner floor (z = FLOOR_Z)
FLOOR_Z = WALL_H
MUZZLE_R = 17.2
MUZZLE_Y = -10.5
MUZZLE_H = 3.6
MUZZLE_F = 1.4         # edge round on the muzzle
NOSE_Y = -5.3
NOSE_R = 5.9
NOSE_H = 3.0           # below the muzzle face
NOSE_F = 1.3
EYE_X = 18.3
EYE_Y = 15.4
EYE_R = 5.75
EYE_H = 1.8
EYE_F = 0.6
IRIS_R = 2.4
IRIS_H = 0.8
IRIS_DX = -0.6
IRIS_DY = -0.6
PUPIL_R = 1.1
PUPIL_H = 0.5
INNER_EAR_R = 9.9     # inner-ear marks: circular segment, flat side to the head
INNER_EAR_CUT = 3.35   # chord distance from the segment's circle centre
INNER_EAR_SHIFT = 0.2  # chord offset from the ear centre (+ = away from head)
INNER_EAR_H = 1.8

# wall arc (in local coords: d = distance inward from the rim, z up)
ARC_UC = (WALL_INSET ** 2 + WALL_H ** 2 + 2 * WALL_H * ARC_DROP) / (2 * WALL_INSET)
ARC_R = math.sqrt(ARC_UC ** 2 + ARC_DROP ** 2)


def wall_d(z, t=0.0):
    """inward distance of the wall surface from the rim outline at height z
    (t = 0 outer skin, t = WALL_T inner skin)."""
    return ARC_UC - math.sqrt((ARC_R - t) ** 2 - (z + ARC_DROP) ** 2)


def waste_profile(wp, t):
    """closed (d, z) region outside the wall skin, drawn on workplane wp."""
    d0 = wall_d(0.0, t)
    dm = wall_d(WALL_H * 0.5, t)
    dh = wall_d(WALL_H, t)
    return (wp.moveTo(-EPS, -EPS).lineTo(d0, -EPS).lineTo(d0, 0)
            .threePointArc((dm, WALL_H * 0.5), (dh, WALL_H))
            .lineTo(dh, WALL_H + EPS).lineTo(-EPS, WALL_H + EPS).close())


def head_lobe(t, z0):
    """solid of revolution for the head (outer skin t=0, cavity t=WALL_T)."""
    R = HEAD_R
    d0 = wall_d(0.0, t)
    dm = wall_d(WALL_H * 0.5, t)
    dh = wall_d(WALL_H, t)
    wp = cq.Workplane("XZ").moveTo(0, z0).lineTo(R - d0, z0)
    if z0 < 0:
        wp = wp.lineTo(R - d0, 0)
    wp = (wp.threePointArc((R - dm, WALL_H * 0.5), (R - dh, WALL_H))
          .lineTo(0, WALL_H).close())
    return wp.revolve(360, (0, 0, 0), (0, 1, 0))


def ear_frame(sx):
    ang = math.radians(-EAR_TILT if sx < 0 else 180.0 + EAR_TILT)
    u = cq.Vector(math.cos(ang), math.sin(ang), 0)       # major axis (towards head)
    v = cq.Vector(-math.sin(ang), math.cos(ang), 0)
    c = cq.Vector(sx * EAR_CX, EAR_CY, 0)
    return c, u, v


def ear_cut_sweep(sx, z0, z1, draw_waste):
    """elliptic ear cylinder (z0..z1) minus a waste profile swept round
    its rim; draw_waste(workplane) draws the (d, z) waste region."""
    c, u, v = ear_frame(sx)
    ang = math.degrees(math.atan2(u.y, u.x))
    cyl = (cq.Workplane("XY").workplane(offset=z0).center(c.x, c.y)
           .ellipse(EAR_A, EAR_B, ang).extrude(z1 - z0))
    path = cq.Wire.makeEllipse(EAR_A, EAR_B, c, cq.Vector(0, 0, 1), u)
    plane = cq.Plane(origin=c + u * EAR_A, xDir=-u, normal=v)
    waste = draw_waste(cq.Workplane(plane)).sweep(
        cq.Workplane().add(path), transition="right")
    return cyl.cut(waste)


def ear_lobe(sx, t, z0):
    """elliptic ear lobe with the same constant wall profile swept round it."""
    return ear_cut_sweep(sx, z0, WALL_H, lambda wp: waste_profile(wp, t))


def plate_outline_solid():
    off = WALL_INSET - BASE_OVERHANG
    p = (cq.Workplane("XY").workplane(offset=WALL_H)
         .circle(HEAD_R - off).extrude(BASE_T))
    for sx in (-1, 1):
        e = ear_cut_sweep(
            sx, WALL_H, WALL_H + BASE_T,
            lambda wp: wp.center(0.5 * (off - EPS), WALL_H + 0.5 * BASE_T)
            .rect(off + EPS, BASE_T + 2 * EPS))
        p = p.union(e)
    return p


outer = head_lobe(0.0, 0.0)
cavity = head_lobe(WALL_T, -EPS)
for sx in (-1, 1):
    outer = outer.union(ear_lobe(sx, 0.0, 0.0))
    cavity = cavity.union(ear_lobe(sx, WALL_T, -EPS))

body = outer.union(plate_outline_solid()).cut(cavity)


def disc(x, y, r, z_top, h, fillet=0.0):
    """round boss hanging down from z_top, optional round on its free edge"""
    d = (cq.Workplane("XY").workplane(offset=z_top)
         .center(x, y).circle(r).extrude(-h))
    if fillet > 0:
        d = d.faces("<Z").edges().fillet(fillet)
    return d


# muzzle with the nose
body = body.union(disc(0, MUZZLE_Y, MUZZLE_R, FLOOR_Z + OVL, MUZZLE_H + OVL, MUZZLE_F))
body = body.union(disc(0, NOSE_Y, NOSE_R, FLOOR_Z - MUZZLE_H + OVL, NOSE_H + OVL, NOSE_F))

# eyes: disc + iris + pupil
for sx in (-1, 1):
    ex, ey = sx * EYE_X, EYE_Y
    body = body.union(disc(ex, ey, EYE_R, FLOOR_Z + OVL, EYE_H + OVL, EYE_F))
    ix, iy = ex + IRIS_DX, ey + IRIS_DY
    body = body.union(disc(ix, iy, IRIS_R, FLOOR_Z - EYE_H + OVL, IRIS_H + OVL))
    body = body.union(disc(ix, iy, PUPIL_R, FLOOR_Z - EYE_H - IRIS_H + OVL, PUPIL_H + OVL))

# inner-ear marks (circular segments, chord facing the head centre)
for sx in (-1, 1):
    c, u, v = ear_frame(sx)
    to_head = (cq.Vector(0, 0, 0) - c).normalized()
    ang = math.degrees(math.atan2(to_head.y, to_head.x))
    chord = c - to_head * INNER_EAR_SHIFT
    w = math.sqrt(INNER_EAR_R ** 2 - INNER_EAR_CUT ** 2)
    seg = (cq.Workplane("XY").workplane(offset=FLOOR_Z + OVL)
           .center(chord.x, chord.y)
           .transformed(rotate=(0, 0, ang + 90.0))
           .moveTo(-w, 0).lineTo(w, 0)
           .threePointArc((0, INNER_EAR_CUT + INNER_EAR_R), (-w, 0)).close()
           .extrude(-(INNER_EAR_H + OVL)))
    body = body.union(seg)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
